"""Cast bracket: an L-shaped extruded profile (thin floor with an end lip, a step up to a
thick base, a radiused bend into an upright arm with a round crown), a raised pad on the
outside of the arm with a filleted counterbore and through hole, and a hole in the floor.
X runs along the base towards the arm, Y across the width, Z up."""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 20.0            # width of the bracket along Y
LIP_T = 1.5         # thickness of the end lip
LIP_H = 10.4        # height of lip top
FLOOR_Z = 6.0       # top of the thin floor
STEP_X = 17.4       # x position of the step in the floor
BASE_Z = 10.4       # top of the thick base
ARM_IN_X = 36.0     # inner face of the upright arm
ARM_OUT_X = 42.6    # outer face of the upright arm
ARM_TOP = 37.5      # top of the arm
R_BL = 3.0          # bottom left corner radius
R_OUT = 10.0        # outer bend radius
R_IN = 10.0         # inner bend radius
R_SMALL = 0.5       # small edge rounds on lip / step

PAD_X = 47.5        # outer face of the raised pad on the arm
HOLE_Z = ARM_TOP - W / 2.0   # centre of arm hole (centre of top round)
CB_R = 4.95         # counterbore radius around arm hole
CB_FLOOR_X = 37.4   # counterbore floor position
CB_BOT_R = 1.6      # fillet at the bottom of the counterbore
ARM_HOLE_R = 1.65   # through hole in the arm
BASE_HOLE_X = 9.45  # hole in the thin floor (centred across the width)
BASE_HOLE_R = 1.62
PAD_FILLET = 1.2   # round on the pad rim and counterbore rim
PAD_FOOT_FILLET = 1.3  # concave blend at the foot of the pad / rim of the bore on the arm face
PAD_LOW_FILLET = 0.5   # round on the lower front corner of the pad
PAD_ARC_CY = -11.95 # lower pad boundary: arc centre (Y, Z) and radius
PAD_ARC_CZ = 23.38
PAD_ARC_R = 9.5
PAD_LINE_Y0 = 1.155 # upper pad boundary line: Y at Z=HOLE_Z+4 and at Z=ARM_TOP+2
PAD_LINE_Y1 = 3.11

VIEW = {"azimuth": 45, "elevation": 26}


def _corner(p0, p1, p2, r):
    """Tangent points and arc midpoint of a corner p1 rounded with radius r."""
    if r <= 0:
        return p1, None, p1
    v1 = (p0[0] - p1[0], p0[1] - p1[1])
    v2 = (p2[0] - p1[0], p2[1] - p1[1])
    l1 = math.hypot(*v1)
    l2 = math.hypot(*v2)
    u1 = (v1[0] / l1, v1[1] / l1)
    u2 = (v2[0] / l2, v2[1] / l2)
    ang = math.acos(max(-1.0, min(1.0, u1[0] * u2[0] + u1[1] * u2[1])))
    t = r / math.tan(ang / 2.0)
    a = (p1[0] + u1[0] * t, p1[1] + u1[1] * t)
    b = (p1[0] + u2[0] * t, p1[1] + u2[1] * t)
    bis = (u1[0] + u2[0], u1[1] + u2[1])
    lb = math.hypot(*bis)
    bis = (bis[0] / lb, bis[1] / lb)
    dc = r / math.sin(ang / 2.0)
    c = (p1[0] + bis[0] * dc, p1[1] + bis[1] * dc)
    m = (c[0] - bis[0] * r, c[1] - bis[1] * r)
    return a, m, b


def rounded_profile(wp, pts, radii):
    """Closed polygon on workplane wp with each corner rounded by its radius (0 = sharp)."""
    n = len(pts)
    corners = [_corner(pts[i - 1], pts[i], pts[(i + 1) % n], radii[i]) for i in range(n)]
    w = wp.moveTo(*corners[0][2])
    for i in range(1, n + 1):
        a, m, b = corners[i % n]
        w = w.lineTo(*a)
        if m is not None:
            w = w.threePointArc(m, b)
    return w.close()


# ---------------- side profile (XZ) extruded along Y ----------------
prof_pts = [
    (0.0, 0.0),
    (ARM_OUT_X, 0.0),
    (ARM_OUT_X, ARM_TOP),
    (ARM_IN_X, ARM_TOP),
    (ARM_IN_X, BASE_Z),
    (STEP_X, BASE_Z),
    (STEP_X, FLOOR_Z),
    (LIP_T, FLOOR_Z),
    (LIP_T, LIP_H),
    (0.0, LIP_H),
]
prof_r = [R_BL, R_OUT, 0.0, 0.0, R_IN, R_SMALL, 0.3, R_SMALL, R_SMALL * 0.8, R_SMALL * 0.8]

body = rounded_profile(cq.Workplane("XZ"), prof_pts, prof_r).extrude(W / 2.0, both=True)

# rounded top of the arm: intersect with a YZ outline (rectangle + half circle)
yz_outline = (
    cq.Workplane("YZ", origin=(-5.0, 0, 0))
    .center(0, HOLE_Z / 2.0 - 1.0)
    .rect(W, HOLE_Z + 2.0)
    .extrude(PAD_X + 10.0)
    .union(
        cq.Workplane("YZ", origin=(-5.0, 0, 0))
        .center(0, HOLE_Z)
        .circle(W / 2.0)
        .extrude(PAD_X + 10.0)
    )
)
body = body.intersect(yz_outline)

# ---------------- raised pad on the outer face of the arm ----------------
class FnSel(cq.Selector):
    """Select objects with an arbitrary predicate."""

    def __init__(self, fn):
        self.fn = fn

    def filter(self, objs):
        return [o for o in objs if self.fn(o)]


def on_x(xv, tol=1e-3):
    def f(e):
        bb = e.BoundingBox()
        return abs(bb.xmin - xv) < tol and abs(bb.xmax - xv) < tol
    return f


# lower boundary of the pad: arc of radius PAD_ARC_R centred outside the -Y face
_a_mid = math.radians(-45.0)
pad_sk = (
    cq.Workplane("YZ", origin=(ARM_OUT_X - 0.5, 0, 0))
    .moveTo(PAD_ARC_CY, PAD_ARC_CZ - PAD_ARC_R)
    .threePointArc(
        (PAD_ARC_CY + PAD_ARC_R * math.cos(_a_mid), PAD_ARC_CZ + PAD_ARC_R * math.sin(_a_mid)),
        (PAD_ARC_CY + PAD_ARC_R, PAD_ARC_CZ),
    )
    .lineTo(0.0, HOLE_Z)
    .lineTo(PAD_LINE_Y0, HOLE_Z + 4.0)
    .lineTo(PAD_LINE_Y1, ARM_TOP + 2.0)
    .lineTo(PAD_ARC_CY - 0.5, ARM_TOP + 2.0)
    .close()
    .extrude(PAD_X - ARM_OUT_X + 0.5)
)
pad = pad_sk.intersect(yz_outline)
body = body.union(pad)

# ---------------- counterbore + hole in the arm ----------------
cb_prof = (
    cq.Workplane("XY", origin=(0, 0, HOLE_Z))
    .moveTo(CB_FLOOR_X, 0)
    .lineTo(CB_FLOOR_X, CB_R - CB_BOT_R)
    .threePointArc(
        (CB_FLOOR_X + CB_BOT_R * (1 - math.sqrt(0.5)), CB_R - CB_BOT_R * (1 - math.sqrt(0.5))),
        (CB_FLOOR_X + CB_BOT_R, CB_R),
    )
    .lineTo(PAD_X + 2.0, CB_R)
    .lineTo(PAD_X + 2.0, 0)
    .close()
    .revolve(360, (0, 0, 0), (1, 0, 0))
)
body = body.cut(cb_prof)


def is_crown_arc(e):
    """Edge lying on the rounded crown of the arm (radius W/2 about the hole axis)."""
    for t in (0.0, 0.25, 0.5, 0.75, 1.0):
        p = e.positionAt(t)
        if abs(math.hypot(p.y, p.z - HOLE_Z) - W / 2.0) > 1e-3:
            return False
    return True


def foot_edge(e):
    bb = e.BoundingBox()
    if not on_x(ARM_OUT_X)(e):
        return False
    if bb.zmin < PAD_ARC_CZ - PAD_ARC_R - 1.0:
        return False
    if abs(bb.ymin - bb.ymax) < 1e-3 and abs(abs(bb.ymin) - W / 2.0) < 1e-3:
        return False
    return not is_crown_arc(e)


def pad_bottom_front_edge(e):
    bb = e.BoundingBox()
    return (
        abs(bb.ymin + W / 2.0) < 1e-3
        and abs(bb.ymax + W / 2.0) < 1e-3
        and abs(bb.xmin - ARM_OUT_X) < 1e-3
        and abs(bb.xmax - PAD_X) < 1e-3
        and bb.zmax < PAD_ARC_CZ - PAD_ARC_R + 1.5
    )


# round the lower corner of the pad where it meets the -Y face
body = body.edges(FnSel(pad_bottom_front_edge)).fillet(PAD_LOW_FILLET)
# blend the foot of the pad and round the rim of the counterbore on the arm face
body = body.edges(FnSel(foot_edge)).fillet(PAD_FOOT_FILLET)
# round the outer rim of the pad (including the counterbore rim on the pad face)
body = body.edges(FnSel(on_x(PAD_X))).fillet(PAD_FILLET)

arm_hole = (
    cq.Workplane("YZ", origin=(ARM_IN_X - 2.0, 0, 0))
    .center(0, HOLE_Z)
    .circle(ARM_HOLE_R)
    .extrude(20.0)
)
body = body.cut(arm_hole)

# ---------------- hole in the floor ----------------
base_hole = (
    cq.Workplane("XY", origin=(0, 0, -1.0))
    .center(BASE_HOLE_X, 0)
    .circle(BASE_HOLE_R)
    .extrude(FLOOR_Z + 2.0)
)
body = body.cut(base_hole)

result = body
